import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
L = 120.0          # overall length (X)
W = 45.0           # overall depth (Y)
H = 37.0           # body height above the lip (Z)
CX = 27.0          # front plan corner arc: tangent point distance from end face
CY = 14.5          # front plan corner arc: meets end face this far behind front
R_FRONT = 11.5     # big top-front round
R_SMALL = 2.0      # small round on end faces / back top edge
R_BACKV = 2.5      # back vertical corner round
T = 3.0            # wall thickness
LIP_H = 1.6        # bottom lip height
LIP_IN = 1.5       # lip inset from outer wall (front and ends)
ARCH_R = 23.9      # arch (cable passage) radius, centred on body bottom
HEX_N = 8
HEX_PITCH = 8.6
HEX_AF = 5.25      # hex across flats (flats face +/-X)
HEX_Y = W / 2 - 14.1
TAB_W = 26.5
TAB_X = 5.4
TAB_DROP = 3.8
BOSS_X = 42.2
BOSS_Y = -3.8
BOSS_D = 12.2
BOSS_HOLE = 4.0

VIEW = {"azimuth": 45, "elevation": 26}

RC = (CX ** 2 + CY ** 2) / (2 * CY)      # plan corner arc radius
CCX = L / 2 - CX                          # corner arc centre x
CCY = -W / 2 + RC                         # corner arc centre y


def plan(off=0.0, back_flush=False, extended=False):
    """Plan outline (XY) offset inward by `off`.
    extended: corner arcs run a full quarter and sides go straight back (used before trimming ends)."""
    hy_f = -W / 2 + off
    hy_b = W / 2 if back_flush else W / 2 - off
    r = RC - off
    m = math.sqrt(0.5)
    if extended:
        ex = CCX + r
        return (cq.Workplane("XY").moveTo(-CCX, hy_f).lineTo(CCX, hy_f)
                .threePointArc((CCX + r * m, CCY - r * m), (ex, CCY))
                .lineTo(ex, hy_b).lineTo(-ex, hy_b).lineTo(-ex, CCY)
                .threePointArc((-CCX - r * m, CCY - r * m), (-CCX, hy_f)).close())
    hx = L / 2 - off
    y_end = CCY - math.sqrt(r ** 2 - (hx - CCX) ** 2)
    a0 = math.atan2(y_end - CCY, hx - CCX)
    am = 0.5 * (a0 - math.pi / 2)
    mid = (CCX + r * math.cos(am), CCY + r * math.sin(am))
    return (cq.Workplane("XY").moveTo(-CCX, hy_f).lineTo(CCX, hy_f)
            .threePointArc(mid, (hx, y_end)).lineTo(hx, hy_b).lineTo(-hx, hy_b)
            .lineTo(-hx, y_end).threePointArc((-mid[0], mid[1]), (-CCX, hy_f)).close())


def rounded_block(off, z0, z1, r_front, r_small, r_back=0.0):
    """Block of the housing shape offset inward by `off`, from z0 up to z1."""
    big = plan(off, extended=True).extrude(z1 - z0).translate((0, 0, z0))
    top = [e for e in big.faces(">Z").edges().vals() if e.Center().y < W / 2 - off - 1]
    big = big.newObject(top).fillet(r_front)
    box = cq.Workplane("XY").box(L - 2 * off, W - 2 * off, z1 - z0 + 2,
                                 centered=(True, True, False)).translate((0, 0, z0 - 1))
    blk = big.intersect(box)
    if r_back > 0:
        blk = blk.edges("|Z").edges(cq.selectors.BoxSelector(
            (-L, W / 2 - off - 0.1, z0 - 1), (L, W / 2 - off + 0.1, z1 + 1))).fillet(r_back)
    if r_small > 0:
        sel = []
        for e in blk.edges().vals():
            c = e.Center()
            bb = e.BoundingBox()
            if bb.zmin < z0 + 0.1:
                continue
            on_end = abs(abs(c.x) - (L / 2 - off)) < 0.05
            on_top_back = bb.zmin > z1 - 0.1 and c.y > W / 2 - off - r_back - 3
            if on_end or on_top_back:
                sel.append(e)
        blk = blk.newObject(sel).fillet(r_small)
    return blk


# ---------------- outer housing ----------------
outer = rounded_block(0.0, 0.0, H, R_FRONT, R_SMALL, R_BACKV)
# lip below the housing: inset on front / ends, flush at the back
lip = plan(LIP_IN, back_flush=True).extrude(LIP_H).translate((0, 0, -LIP_H))
lip = lip.edges("|Z").edges(">Y").fillet(1.0)
body = outer.union(lip)

# ---------------- hollow it out ----------------
cavity = rounded_block(T, -LIP_H - 1.0, H - T, R_FRONT - T, 0.0)
body = body.cut(cavity)

# ---------------- arch (cable passage) through the front wall ----------------
arch = (cq.Workplane("XZ").circle(ARCH_R).extrude(-(T + 2))
        .translate((0, -W / 2 - 1, 0)))
arch = arch.union(cq.Workplane("XY").box(2 * ARCH_R, T + 2, LIP_H + 2, centered=(True, False, False))
                  .translate((0, -W / 2 - 1, -LIP_H - 1)))
body = body.cut(arch)

# ---------------- cross rib over the arch (hides the hex holes from below) ----------------
RIB_Y0, RIB_Y1 = -4.0, -2.0
RIB_X = 28.5
RIB_Z0 = 19.0
rib = (cq.Workplane("XY").box(2 * RIB_X, RIB_Y1 - RIB_Y0, H - T - RIB_Z0 + 1.0, centered=(True, False, False))
       .translate((0, RIB_Y0, RIB_Z0)))
rib = rib.cut(cq.Workplane("XZ").circle(ARCH_R).extrude(-20.0).translate((0, RIB_Y0 - 5, 0)))
body = body.union(rib)
# solid block behind the rib, under the front edge of the hex holes
BLK_Y1 = 5.2
BLK_Z0 = 20.8
blk = (cq.Workplane("XY").box(2 * RIB_X, BLK_Y1 - RIB_Y1, H - T - BLK_Z0 + 1.0, centered=(True, False, False))
       .translate((0, RIB_Y1, BLK_Z0)))
body = body.union(blk)

# ---------------- PCB ledge along the back wall ----------------
LEDGE_X0, LEDGE_X1 = -38.0, 44.5
yb = W / 2 - T + 0.5
ledge_prof = [(yb, 8.4), (13.4, 8.4), (13.4, 10.9), (10.6, 10.9), (10.6, 8.4), (9.7, 8.4),
              (9.0, 9.1), (9.0, 10.7), (14.5, 16.2), (14.5, 20.8), (yb, 20.8)]
ledge = (cq.Workplane("YZ").polyline(ledge_prof).close().extrude(LEDGE_X1 - LEDGE_X0)
         .translate((LEDGE_X0, 0, 0)))
body = body.union(ledge)
# narrow rear part of the ledge runs on towards the screw bosses
LEDGE_EXT_X0, LEDGE_EXT_X1 = -48.0, 50.0
LEDGE_EXT_Y = 16.0
ext = (cq.Workplane("XY").box(LEDGE_EXT_X1 - LEDGE_EXT_X0, yb - LEDGE_EXT_Y, 20.8 - 8.4, centered=False)
       .translate((LEDGE_EXT_X0, LEDGE_EXT_Y, 8.4)))
body = body.union(ext)
# support feet under the ends of the ledge, flush with the housing bottom
for (x0, x1, y0) in ((-48.0, -39.0, 11.4), (35.0, LEDGE_X1, 7.5)):
    foot = (cq.Workplane("XY").box(x1 - x0, yb - y0, 8.9, centered=False)
            .translate((x0, y0, 0.0)))
    body = body.union(foot)
# locating slot in the bottom of the left foot
slot = cq.Workplane("XY").box(7.0, 1.6, 3.5, centered=(True, True, False)).translate((-43.5, 13.6, -0.5))
body = body.cut(slot)

# ---------------- screw bosses ----------------
for sx in (-1, 1):
    boss = (cq.Workplane("XY").center(sx * BOSS_X, BOSS_Y).circle(BOSS_D / 2)
            .extrude(H - T + 0.5))
    body = body.union(boss)
    hole = (cq.Workplane("XY").center(sx * BOSS_X, BOSS_Y).circle(BOSS_HOLE / 2)
            .extrude(H - T - 4).translate((0, 0, -1)))
    body = body.cut(hole)

# ---------------- locating tab on the back edge ----------------
tab_o = (cq.Workplane("XY").box(TAB_W, 1.5, TAB_DROP, centered=(True, False, False))
         .translate((TAB_X, W / 2 - 1.5, -LIP_H - TAB_DROP)))
tab_i = (cq.Workplane("XY").box(TAB_W - 2.6, 1.5, TAB_DROP, centered=(True, False, False))
         .translate((TAB_X, W / 2 - 3.0, -LIP_H - TAB_DROP)))
body = body.union(tab_o).union(tab_i)

# ---------------- hexagonal holes through the top ----------------
hex_d = HEX_AF * 2 / math.sqrt(3)          # across corners
hex_pts = [((i - (HEX_N - 1) / 2) * HEX_PITCH, HEX_Y) for i in range(HEX_N)]
hex_cut = None
for (x, y) in hex_pts:
    h = (cq.Workplane("XY").polygon(6, hex_d).extrude(T + 2)
         .rotate((0, 0, 0), (0, 0, 1), 30).translate((x, y, H - T - 1)))
    hex_cut = h if hex_cut is None else hex_cut.union(h)
body = body.cut(hex_cut)

result = body
